import math
import cadquery as cq

# Toy-car wheel: treaded tyre on a five-spoke dished rim with an axle boss underneath.
# Wheel axis = Z, outer (spoke) face up, open cup underneath.

# ---------------- driving dimensions (mm) ----------------
D_OUT = 65.0            # outer diameter over the tread blocks
H = 29.0                # overall width of the wheel (along Z)
ZC = H / 2.0            # mid plane of the tyre
TREAD_H = 1.0           # height of the tread blocks on the crown
R_OUT = D_OUT / 2.0
R_BASE = R_OUT - TREAD_H    # tyre carcass radius between the blocks
R_BORE = 23.9           # bore of the tyre / outside of the rim barrel
R_CREST = 26.1          # radius of the crest of the tyre side faces
CROWN_ENV_R = 62.5      # crown rows: block tops follow a slightly crowned arc
ENV_Z = 8.3             # (from mid plane) split between crown and shoulder block envelopes
SH_ENV = [(32.2, 8.8), (31.7, 11.0), (29.8, 13.1)]   # shoulder rows: block tops through these

# rim / spoke disc
R_WELL = 19.6           # radius of the rim well above the spokes
Z_RIM = 27.0            # top of the rim flange
RIM_LIP_FIL = 2.0       # rounding of the rim lip into the well
RIM_OUT_FIL = 1.9       # rounding of the rim flange towards the tyre
Z_DISC_BOT = 14.9       # underside of the spoke disc
Z_SPOKE_OUT = 23.7      # spoke top at the well wall
SPOKE_SLOPE = 0.28      # spokes rise towards the hub (dished)
N_SPOKES = 5
WIN_R_IN = 9.7          # inner end of the windows (from the wheel axis)
WIN_HALF = 31.0         # half angle between the straight flanks of a window
WIN_FIL = 6.9           # round at the inner end of the windows
WIN_EDGE_FIL = 0.8      # rounding of the window edges on the spoke tops

# hub
R_CRATER = 7.0          # central pit in the hub
CRATER_FIL = 2.5        # rounded lip of the pit
Z_CRATER = 21.0         # pit floor
R_BUTTON = 4.7          # domed button in the pit
Z_BUTTON = 24.8         # top of the dome
BUTTON_DOME = 3.2       # height of the rounded (spline-profile) dome
R_HUB = 4.85            # axle boss below the disc
Z_HUB_BOT = 2.4
R_HUB_GROOVE = 6.1      # relief groove round the boss under the disc
HUB_GROOVE_D = 1.5
SLOT_L = 4.3            # axle hole (rectangular)
SLOT_W = 2.5
SLOT_DEPTH = 8.0

# tread pattern
N_BLOCKS = 30           # blocks round the circumference (per row)
BLOCK_W = 4.3           # circumferential width of a block
ROW2 = (1.1, 7.5)       # crown row, z range above the mid plane
ROW1 = (8.8, 13.1)      # shoulder row, z range above the mid plane
SLANT2 = 0.333          # tangential shift per mm of z, crown rows
SLANT1 = 0.26           # shoulder rows (opposite hand -> zig-zag)

SEAM_ANGLE = 225.0      # where the revolve seams of the round faces sit (least visible spot)


def arc_mid(c, r, p0, p1):
    """midpoint on circle (centre c, radius r) between p0 and p1 (short arc)"""
    a0 = math.atan2(p0[1] - c[1], p0[0] - c[0])
    a1 = math.atan2(p1[1] - c[1], p1[0] - c[0])
    d = (a1 - a0 + math.pi) % (2 * math.pi) - math.pi
    am = a0 + d / 2.0
    return (c[0] + r * math.cos(am), c[1] + r * math.sin(am))


def revolve_z(wp):
    """full revolve of an XZ-plane section about Z; the seam is turned to SEAM_ANGLE"""
    return wp.revolve(360, (0, 0, 0), (0, 1, 0)).rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)


# ---------------- tyre carcass (one revolved section) ----------------
# bore (cylinder) -> side face (one round arc over the crest into the shoulder) -> crown (cylinder)
r_sh = R_BASE - R_CREST                   # shoulder / side-face round radius
z_sh = ZC - r_sh                          # (from mid plane) top of the cylindrical crown
z_edge = z_sh + math.sqrt(r_sh ** 2 - (R_CREST - R_BORE) ** 2)   # bore edge height
a_edge = math.atan2(z_edge - z_sh, R_BORE - R_CREST)
a_m = a_edge / 2.0
m_top = (R_CREST + r_sh * math.cos(a_m), ZC + z_sh + r_sh * math.sin(a_m))
m_bot = (m_top[0], 2 * ZC - m_top[1])
carcass = revolve_z(
    cq.Workplane("XZ")
    .moveTo(R_BORE, ZC - z_edge)
    .lineTo(R_BORE, ZC + z_edge)
    .threePointArc(m_top, (R_BASE, ZC + z_sh))
    .lineTo(R_BASE, ZC - z_sh)
    .threePointArc(m_bot, (R_BORE, ZC - z_edge))
    .close())

# envelope of the block tops: a flat crown arc for the two middle rows and a shoulder arc
# (falling away towards the side faces) for the outer rows; joined inside the groove


def circle3(p1, p2, p3):
    (ax, ay), (bx, by), (cx, cy) = p1, p2, p3
    d = 2 * (ax * (by - cy) + bx * (cy - ay) + cx * (ay - by))
    ux = ((ax * ax + ay * ay) * (by - cy) + (bx * bx + by * by) * (cy - ay) + (cx * cx + cy * cy) * (ay - by)) / d
    uy = ((ax * ax + ay * ay) * (cx - bx) + (bx * bx + by * by) * (ax - cx) + (cx * cx + cy * cy) * (bx - ax)) / d
    return (ux, uy), math.hypot(ax - ux, ay - uy)


sh_c, sh_r = circle3(*SH_ENV)
sh_top = sh_c[1] + sh_r                          # (from mid plane) top of the shoulder arc
r_sh_split = sh_c[0] + math.sqrt(sh_r ** 2 - (ENV_Z - sh_c[1]) ** 2)
cr_c = (R_OUT - CROWN_ENV_R, 0.0)
r_cr_split = cr_c[0] + math.sqrt(CROWN_ENV_R ** 2 - ENV_Z ** 2)
m_sh = arc_mid(sh_c, sh_r, (r_sh_split, ENV_Z), (sh_c[0], sh_top))
envelope = revolve_z(
    cq.Workplane("XZ")
    .moveTo(0, ZC - sh_top)
    .lineTo(sh_c[0], ZC - sh_top)
    .threePointArc((m_sh[0], ZC - m_sh[1]), (r_sh_split, ZC - ENV_Z))
    .lineTo(r_cr_split, ZC - ENV_Z)
    .threePointArc((R_OUT, ZC), (r_cr_split, ZC + ENV_Z))
    .lineTo(r_sh_split, ZC + ENV_Z)
    .threePointArc((m_sh[0], ZC + m_sh[1]), (sh_c[0], ZC + sh_top))
    .lineTo(0, ZC + sh_top)
    .close())

# ---------------- tread blocks ----------------


def make_block(pts, r_in):
    """parallelogram block (tangential s, z) on the -Y side, trimmed by the envelope"""
    prism = (cq.Workplane("XZ").workplane(offset=r_in)
             .polyline(pts).close().extrude(R_OUT + 2.0 - r_in))
    return prism.intersect(envelope)


# crown row (upper half) "/" : top edge shifted towards +theta
s2_top = -BLOCK_W / 2.0 + SLANT2 * (ROW2[1] - ROW2[0]) / 2.0
s2_bot = s2_top - SLANT2 * (ROW2[1] - ROW2[0])
row2 = [(s2_bot, ZC + ROW2[0]), (s2_bot + BLOCK_W, ZC + ROW2[0]),
        (s2_top + BLOCK_W, ZC + ROW2[1]), (s2_top, ZC + ROW2[1])]
# shoulder row (upper half) "\" : its lower edge continues from the crown-row top edge
s1_bot = s2_top
s1_top = s1_bot - SLANT1 * (ROW1[1] - ROW1[0])
row1 = [(s1_bot, ZC + ROW1[0]), (s1_bot + BLOCK_W, ZC + ROW1[0]),
        (s1_top + BLOCK_W, ZC + ROW1[1]), (s1_top, ZC + ROW1[1])]


def mirror_pts(pts):
    return [(s, 2 * ZC - z) for (s, z) in pts][::-1]


rows = [row1, row2, mirror_pts(row2), mirror_pts(row1)]
# radius where each block prism starts (well inside the carcass)
r_inner = [R_CREST - 0.1, R_BASE - 0.7, R_BASE - 0.7, R_CREST - 0.1]
# blocks are trimmed to the carcass surface so that they can be glued on (fast, exact boolean)
blocks_src = [make_block(p, ri).cut(carcass).val() for p, ri in zip(rows, r_inner)]
block_solids = []
for k in range(N_BLOCKS):
    ang = 360.0 / N_BLOCKS * k
    for b in blocks_src:
        block_solids.append(b.rotate((0, 0, 0), (0, 0, 1), ang))


def glue_fuse(base, tools):
    """boolean union of solids that only touch `base` along shared faces (glue mode)"""
    from OCP.BRepAlgoAPI import BRepAlgoAPI_Fuse
    from OCP.TopTools import TopTools_ListOfShape
    from OCP.BOPAlgo import BOPAlgo_GlueShift
    args, tls = TopTools_ListOfShape(), TopTools_ListOfShape()
    args.Append(base.wrapped)
    for t in tools:
        tls.Append(t.wrapped)
    op = BRepAlgoAPI_Fuse()
    op.SetArguments(args)
    op.SetTools(tls)
    op.SetGlue(BOPAlgo_GlueShift)
    op.SetRunParallel(True)
    op.Build()
    if not op.IsDone():
        raise RuntimeError("glue fuse failed")
    return cq.Shape.cast(op.Shape())


try:
    tire_shape = glue_fuse(carcass.val(), block_solids)
    if len(tire_shape.Solids()) != 1 or not tire_shape.isValid():
        raise RuntimeError("glue fuse gave a bad solid")
    tire = cq.Workplane("XY").add(tire_shape.Solids()[0])
except Exception:
    tire = carcass.union(cq.Workplane("XY").add(cq.Compound.makeCompound(block_solids)))

# ---------------- rim, spoke disc and hub (revolved sections) ----------------


def z_cone(r):
    return Z_SPOKE_OUT + SPOKE_SLOPE * (R_WELL - r)


s = SPOKE_SLOPE
nrm = math.sqrt(1 + s * s)
zc0 = z_cone(R_CRATER)
f = CRATER_FIL
cf = (R_CRATER + f, zc0 - s * f - f * nrm)            # pit lip round: centre
t_wall = (R_CRATER, cf[1])
t_cone = (cf[0] + f * s / nrm, cf[1] + f / nrm)
m_lip = arc_mid(cf, f, t_cone, t_wall)
lf = RIM_LIP_FIL
l_c = (R_WELL + lf, Z_RIM - lf)
m_rim = arc_mid(l_c, lf, (R_WELL + lf, Z_RIM), (R_WELL, Z_RIM - lf))
of = RIM_OUT_FIL
r_barrel = R_BORE + 0.3                     # rim barrel, sunk slightly into the tyre bore
o_c = (r_barrel - of, Z_RIM - of)
m_out = arc_mid(o_c, of, (r_barrel, Z_RIM - of), (r_barrel - of, Z_RIM))

R_DISC = R_WELL + 0.6                       # disc runs into the rim ring (hidden overlap)
disc = revolve_z(
    cq.Workplane("XZ")
    .moveTo(0, Z_HUB_BOT)
    .lineTo(R_HUB, Z_HUB_BOT)
    .lineTo(R_HUB, Z_DISC_BOT + HUB_GROOVE_D)
    .lineTo(R_HUB_GROOVE, Z_DISC_BOT + HUB_GROOVE_D)
    .lineTo(R_HUB_GROOVE, Z_DISC_BOT)
    .lineTo(R_DISC, Z_DISC_BOT)
    .lineTo(R_DISC, z_cone(R_DISC))
    .lineTo(*t_cone)
    .threePointArc(m_lip, t_wall)
    .lineTo(R_CRATER, Z_CRATER)
    .lineTo(R_BUTTON, Z_CRATER)
    .lineTo(R_BUTTON, Z_BUTTON - BUTTON_DOME)
    .spline([(0, Z_BUTTON)], tangents=[(0, 1), (-1, 0)], includeCurrent=True)
    .close())

rim = revolve_z(
    cq.Workplane("XZ")
    .moveTo(R_WELL, Z_DISC_BOT)
    .lineTo(r_barrel, Z_DISC_BOT)
    .lineTo(r_barrel, Z_RIM - of)
    .threePointArc(m_out, (r_barrel - of, Z_RIM))
    .lineTo(R_WELL + lf, Z_RIM)
    .threePointArc(m_rim, (R_WELL, Z_RIM - lf))
    .close())

# windows between the spokes: two straight flanks (WIN_HALF either side of the window
# axis), a round at the inner end and the well wall as outer boundary
sa, ca = math.sin(math.radians(WIN_HALF)), math.cos(math.radians(WIN_HALF))
c_y = WIN_R_IN + WIN_FIL                      # centre of the inner round
apex = c_y - WIN_FIL / sa                     # where the two flanks would meet
t_f = (c_y - apex) * ca                       # flank length from apex to the round
r_wo = R_WELL + 0.3                           # windows end inside the rim ring
t_out = -apex * ca + math.sqrt((apex * ca) ** 2 - apex ** 2 + r_wo ** 2)
w_tr = (t_f * sa, apex + t_f * ca)
w_er = (t_out * sa, apex + t_out * ca)
cut_tools = []
for k in range(N_SPOKES):
    win = (cq.Workplane("XY").workplane(offset=Z_DISC_BOT - 1.0)
           .moveTo(-w_tr[0], w_tr[1])
           .threePointArc((0.0, WIN_R_IN), w_tr)
           .lineTo(*w_er)
           .threePointArc((0.0, r_wo), (-w_er[0], w_er[1]))
           .close()
           .extrude(H + 2.0 - Z_DISC_BOT)
           .val().rotate((0, 0, 0), (0, 0, 1), 360.0 / N_SPOKES * k))
    cut_tools.append(win)
# axle hole
cut_tools.append(cq.Workplane("XY").workplane(offset=Z_HUB_BOT - 0.1)
                 .rect(SLOT_L, SLOT_W).extrude(SLOT_DEPTH).val())
disc = disc.cut(cq.Workplane("XY").add(cq.Compound.makeCompound(cut_tools)))

wheel = disc.union(rim)


def is_window_top(e):
    """edges where the window walls meet the spoke tops"""
    bb = e.BoundingBox()
    if bb.zmin < Z_DISC_BOT + 3.0 or bb.zlen > 6.0:
        return False
    rs = [math.hypot(p.x, p.y) for p in (e.positionAt(t) for t in (0.0, 0.25, 0.5, 0.75, 1.0))]
    if max(rs) - min(rs) < 0.05:                # circles about the wheel axis
        return False
    return min(rs) > WIN_R_IN - 1.0 and max(rs) < R_WELL + 0.1


try:
    wheel = cq.Workplane("XY").add(
        wheel.val().fillet(WIN_EDGE_FIL, [e for e in wheel.val().Edges() if is_window_top(e)]))
except Exception:
    pass

fused = tire.union(wheel).val()
result = cq.Workplane("XY").add(fused.Solids()[0] if len(fused.Solids()) == 1 else fused)

VIEW = {"azimuth": 45, "elevation": 26}
